"""1x1 gridfinity-style storage bin, 4 height units, with a front scoop.

Square cup with rounded vertical corners, thin walls, a solid base block that
ends in a stacking foot (45deg chamfer / straight band / small 45deg chamfer),
flat underside, and an interior whose floor-to-front-wall junction is a large
radius "scoop" so small parts can be slid out.
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 41.5           # outer width of the square body (X and Y)
R = 3.75           # outer vertical corner radius
H_TOTAL = 28.0     # overall height (4 x 7 mm units)
C_BOT = 0.8        # small 45deg chamfer at the very bottom of the foot
H_FOOT = 1.8       # straight band of the foot
C_TOP = 2.15       # 45deg chamfer from the foot up to the outer wall
T = 1.0            # wall thickness
FLOOR = 7.0        # interior floor height (= top of the solid base block)
RI = R - T         # inner vertical corner radius, also floor fillet radius
RS = 11.5          # scoop radius between floor and front (-Y) inner wall

Z_CH = C_BOT + H_FOOT          # height where the big chamfer starts

VIEW = {"azimuth": 45, "elevation": 26}


def rrect_prism(w, r, z0, h):
    """Square prism with rounded vertical corners, from z0 up by h."""
    return (cq.Workplane("XY").workplane(offset=z0)
            .sketch().rect(w, w).vertices().fillet(r).finalize()
            .extrude(h))


# ---------------- solid base block with stacking foot ----------------
base = (rrect_prism(W, R, Z_CH, FLOOR - Z_CH)
        .faces("<Z").edges().chamfer(C_TOP))
WF = W - 2 * C_TOP                                   # foot width
foot = (rrect_prism(WF, R - C_TOP, 0.0, Z_CH)
        .faces("<Z").edges().chamfer(C_BOT))
base = base.union(foot, clean=True)

# ---------------- wall block (kept as its own face band -> seam at FLOOR) ----
walls = rrect_prism(W, R, FLOOR, H_TOTAL - FLOOR)
outer = base.union(walls, clean=False)

# ---------------- interior pocket with the front scoop ----------------
WI = W - 2 * T                    # inner width
ZT = H_TOTAL + 2.0                # pocket tool sticks out above the rim
y0, y1 = -WI / 2, WI / 2
prof = (cq.Workplane("YZ")
        .moveTo(y0, ZT)
        .lineTo(y0, FLOOR + RS)
        .radiusArc((y0 + RS, FLOOR), -RS)   # quarter round scoop
        .lineTo(y1, FLOOR)
        .lineTo(y1, ZT)
        .close()
        .extrude(WI / 2, both=True))


def _round_me(e):
    """Edges of the pocket tool that get the RI round: everything except
    the top face edges and the two tangent seams of the scoop."""
    bb = e.BoundingBox()
    if bb.zmin > ZT - 0.1:                   # edges on the top face
        return False
    if e.geomType() == "LINE" and bb.xlen > WI - 0.1:
        # lines running along X: only the floor / back-wall edge is sharp
        return bb.ymin > y1 - 0.1
    return True


tool = prof.val()
pocket = tool.fillet(RI, [e for e in tool.Edges() if _round_me(e)])

result = outer.cut(pocket, clean=False)
